import cadquery as cq

# ---------------------------------------------------------------------------
# Fixture frame: a flat base grid of ribbed bars, four tall uprights standing
# on the ends of two Y rails, low end posts on the long cross bar, a slotted
# front plate, a chamfered gusset plate, two hole plates on the left rail and
# a set of clip blocks on the right-hand outrigger.
# Units: mm.  X = long cross bar, Y = rail direction (depth), Z = up.
# ---------------------------------------------------------------------------

# ---- overall ----
LX = 236.75                 # length of the long X bar (overall X)
LY = 172.4                  # length of the two Y rails (overall Y)

# ---- base bar section ----
T_FL = 6.1                  # flange (base plate) height
T_RIB = 9.3                 # top of the raised ribs

# long X bar: L-section (flange + rib on its back half)
XB_Y0, XB_Y1 = 82.25, 94.65
XB_RIB_Y0 = 88.65

# Y rails: T-section (flange + centre rib)
RAIL_W = 15.3
RAIL_XC = (85.3, 155.1)                 # rail centre lines (left, right)
RIB_W = 5.8
RL0, RL1 = RAIL_XC[0] - RAIL_W / 2, RAIL_XC[0] + RAIL_W / 2
RR0, RR1 = RAIL_XC[1] - RAIL_W / 2, RAIL_XC[1] + RAIL_W / 2

# ---- feet / tall uprights ----
FOOT_L = 11.8               # foot length at each rail end
BUMP_W, BUMP_Y0, BUMP_Y1, BUMP_H = 5.8, 2.9, 5.75, 3.1
POST_Y0, POST_Y1 = 5.4, 11.8            # upright thickness band (front ones)
POST_H = 103.0
POST_RA, POST_RB = 6.0, 3.6             # elliptical round of the outer top edge
HOLE_R = 2.4
CB_R, CB_D = 4.9, 2.0                   # counterbore on the outer faces
HOLE_Z_FRONT = (69.75,)
HOLE_Z_BACK = (70.0, 31.0)

# ---- end posts of the X bar ----
EP_T = 6.0
EP_H = 62.0
EP_RA, EP_RB = 5.6, 3.4

# ---- small tab with square hole ----
TAB = (8.0, 16.8, 74.5, 83.65, 15.8)    # x0, x1, y0, y1, height
TAB_HOLE = 2.0

# ---- hole plates on the left rail ----
PL_X0, PL_X1 = RL0, RL0 + 6.5
PL_H = 62.0
PL_A_Y = (POST_Y1, 30.7, 24.5)          # y0, y1, hole y
PL_B_Y = (93.0, 109.3, 99.3)
PL_B_R = 6.5                            # rounded top corner
PL_HOLE_R = 2.5
PL_HOLE_Z = (54.5, 38.7)

# ---- slotted front plate ----
FR_Y0, FR_Y1 = 9.25, 15.85              # cross flange carrying the plate
SP_X0, SP_X1 = 97.95, 144.0
SP_Y0, SP_Y1 = 9.25, 13.25
SP_H = 38.75
SLOT_X0, SLOT_X1 = 100.5, 140.5
SLOT_H, SLOT_D = 3.4, 2.0
SLOT_Z = (33.75, 19.25)
SP_HOLE_R, SP_HOLE_Z = 3.5, 26.5
PIN_R, PIN_DX = 0.9, (-15.5, 14.5)

# ---- gusset plate ----
G_X0, G_X1 = 169.2, 175.3
G_PROFILE = [(24.9, 0), (24.9, 68.0), (64.9, 68.0), (64.9, 46.8),
             (40.7, 31.4), (40.7, 0)]   # (y, z) outline
G_HOLES_Y, G_HOLE_Z = (35.9, 57.7), 61.8
G_CB_R, G_CB_D = 4.5, 1.6

# ---- right outrigger ----
OR_X0, OR_X1 = 200.0, 206.0             # outrigger rail
OR_Y0, OR_Y1 = 28.6, 130.2
CLIP_H = 30.9


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def round_top(solid, along, pos, outer_dir, top, length_rng, ra, rb):
    """Elliptical round of the top outer edge of a post.
    along: 'X' or 'Y' (edge direction); pos: coordinate of the outer face;
    outer_dir: -1 if the outer face is on the low side, +1 otherwise."""
    l0, l1 = length_rng
    c = pos - outer_dir * ra
    lo, hi = sorted((pos, c))
    if along == "X":
        corner = box(l0 - 1, l1 + 1, lo, hi, top - rb, top + 1)
        ell = (cq.Workplane("YZ", origin=(l0 - 2, 0, 0)).center(c, top - rb)
               .ellipse(ra, rb).extrude(l1 - l0 + 4))
    else:
        corner = box(lo, hi, l0 - 1, l1 + 1, top - rb, top + 1)
        ell = (cq.Workplane("XZ", origin=(0, l0 - 2, 0)).center(c, top - rb)
               .ellipse(ra, rb).extrude(-(l1 - l0 + 4)))
    return solid.cut(corner.cut(ell))


# ======================= base grid =======================
part = box(0, RR1, XB_Y0, XB_Y1, 0, T_FL)                           # X bar
part = part.union(box(RR1, OR_X0, XB_RIB_Y0, XB_Y1, 0, T_FL))
part = part.union(box(OR_X0, LX, XB_Y0, XB_Y1, 0, T_FL))
part = part.union(box(0, RR1, XB_RIB_Y0, XB_Y1, T_FL, T_RIB))       # X bar rib

for xc in RAIL_XC:                                                  # Y rails
    part = part.union(box(xc - RAIL_W / 2, xc + RAIL_W / 2, 0, LY, 0, T_FL))
    part = part.union(box(xc - RIB_W / 2, xc + RIB_W / 2,
                          FOOT_L, LY - FOOT_L, T_FL, T_RIB))

part = part.union(box(RL1, RR0, FR_Y0, FR_Y1, 0, T_FL))             # front flange

# right outrigger rail and its cross stubs
part = part.union(box(OR_X0, OR_X1, OR_Y0, OR_Y1, 0, T_FL))
part = part.union(box(RR1, 229.5, 34.6, 40.4, 0, T_FL))
part = part.union(box(RR1, OR_X0, 114.8, 120.6, 0, T_FL))
part = part.union(box(OR_X0, 229.2, 124.1, OR_Y1, 0, T_FL))

# ======================= feet and tall uprights =======================
for xc in RAIL_XC:
    x0, x1 = xc - RAIL_W / 2, xc + RAIL_W / 2
    for back in (False, True):
        if back:
            fy0, fy1 = LY - FOOT_L, LY
            py0, py1 = LY - POST_Y1, LY - POST_Y0
            by0, by1 = LY - BUMP_Y1, LY - BUMP_Y0
            outer, odir, zs = py1, 1, HOLE_Z_BACK
        else:
            fy0, fy1 = 0, FOOT_L
            py0, py1 = POST_Y0, POST_Y1
            by0, by1 = BUMP_Y0, BUMP_Y1
            outer, odir, zs = py0, -1, HOLE_Z_FRONT
        part = part.union(box(x0, x1, fy0, fy1, 0, T_FL))                     # foot
        part = part.union(box(xc - BUMP_W / 2, xc + BUMP_W / 2, by0, by1,
                              T_FL, T_FL + BUMP_H))                           # locator
        post = box(x0, x1, py0, py1, 0, POST_H)
        post = round_top(post, "X", outer, odir, POST_H, (x0, x1), POST_RA, POST_RB)
        part = part.union(post)
        for z in zs:        # through holes (Y) with counterbore on the outer face
            part = part.cut(cq.Workplane("XZ", origin=(0, (py0 + py1) / 2, 0))
                            .center(xc, z).circle(HOLE_R).extrude(10, both=True))
            part = part.cut(cq.Workplane("XZ", origin=(0, outer, 0))
                            .center(xc, z).circle(CB_R).extrude(odir * CB_D))

# ======================= end posts of the X bar =======================
ep_l = box(0, EP_T, XB_Y0, XB_Y1, 0, EP_H)
ep_l = round_top(ep_l, "Y", 0, -1, EP_H, (XB_Y0, XB_Y1), EP_RA, EP_RB)
ep_r = box(LX - EP_T, LX, XB_Y0, XB_Y1, 0, EP_H)
ep_r = round_top(ep_r, "Y", LX, 1, EP_H, (XB_Y0, XB_Y1), EP_RA, EP_RB)
part = part.union(ep_l).union(ep_r)

# small tab with a square through hole near the left end
tx0, tx1, ty0, ty1, th = TAB
tab = box(tx0, tx1, ty0, ty1, 0, th)
tcx, tcy = (tx0 + tx1) / 2, (ty0 + ty1) / 2
tab = tab.cut(box(tcx - TAB_HOLE / 2, tcx + TAB_HOLE / 2,
                  tcy - TAB_HOLE / 2, tcy + TAB_HOLE / 2, -1, th + 1))
part = part.union(tab)

# ======================= hole plates on the left rail =======================
for (y0, y1, yh), rounded in ((PL_A_Y, False), (PL_B_Y, True)):
    pl = box(PL_X0, PL_X1, y0, y1, 0, PL_H)
    if rounded:
        pl = pl.edges("|X").edges(">Z").edges(">Y").fillet(PL_B_R)
    for z in PL_HOLE_Z:
        pl = pl.cut(cq.Workplane("YZ", origin=(PL_X0 - 1, 0, 0))
                    .center(yh, z).circle(PL_HOLE_R).extrude(PL_X1 - PL_X0 + 2))
    part = part.union(pl)

# ======================= slotted front plate =======================
sp = box(SP_X0, SP_X1, SP_Y0, SP_Y1, 0, SP_H)
spc = (SP_X0 + SP_X1) / 2
for zc in SLOT_Z:                                   # blind slots in the front face
    sp = sp.cut(box(SLOT_X0, SLOT_X1, SP_Y0 - 1, SP_Y0 + SLOT_D,
                    zc - SLOT_H / 2, zc + SLOT_H / 2))
    for dx in PIN_DX:                               # small pin holes at slot ends
        sp = sp.cut(cq.Workplane("XZ").center(spc + dx, zc)
                    .circle(PIN_R).extrude(50, both=True))
sp = sp.cut(cq.Workplane("XZ").center(spc, SP_HOLE_Z)
            .circle(SP_HOLE_R).extrude(50, both=True))
part = part.union(sp)

# ======================= gusset plate =======================
gus = (cq.Workplane("YZ", origin=(G_X0, 0, 0))
       .polyline(G_PROFILE).close()
       .extrude(G_X1 - G_X0))
for yh in G_HOLES_Y:
    gus = gus.cut(cq.Workplane("YZ", origin=(G_X0 - 1, 0, 0))
                  .center(yh, G_HOLE_Z).circle(HOLE_R).extrude(G_X1 - G_X0 + 2))
    gus = gus.cut(cq.Workplane("YZ", origin=(G_X1 - G_CB_D, 0, 0))
                  .center(yh, G_HOLE_Z).circle(G_CB_R).extrude(5))
part = part.union(gus)

# ======================= clip blocks =======================
clips = [
    (G_X0, G_X1, XB_Y0, XB_Y1),                 # A  on the X bar
    (G_X0, G_X1, 109.8, 120.6),                 # B  L-shaped
    (G_X0, 185.6, 114.8, 120.6),
    (OR_X0, OR_X1, XB_Y0, XB_Y1),               # C  on the X bar / outrigger crossing
    (OR_X0, 206.5, OR_Y0, 41.0),                # D  L-shaped, front of outrigger
    (OR_X0, 212.9, OR_Y0, 34.6),
    (221.7, 229.5, OR_Y0, 34.6),                # E
    (G_X0, 185.0, 18.3, 24.9),                  # F  in front of the gusset
    (OR_X0, OR_X1, 111.3, OR_Y1),               # G  L-shaped, back of outrigger
    (OR_X0, 211.0, 124.1, OR_Y1),
    (220.5, 229.2, 124.1, OR_Y1),               # H
]
for x0, x1, y0, y1 in clips:
    part = part.union(box(x0, x1, y0, y1, 0, CLIP_H))

# centre the part on the origin in X / Y, base on Z = 0
result = part.translate((-LX / 2, -LY / 2, 0))

VIEW = {"azimuth": 45, "elevation": 26}
